import math
import cadquery as cq

# ---------------- driving dimensions (mm) ----------------
R = 100.0          # base disk radius
T = 5.0            # base disk thickness
EDGE_CH = 2.0      # chamfer on disk top edge

RING_RO = 56.0     # tower ring outer radius
RING_RI = 45.0     # tower ring inner radius (bore)
RIM_FILLET = 3.0   # round-over of the tower rim
BASE_FILLET = 4.0  # fillet where the tower meets the disk
NECK_A = 50.0      # angle where the neck blend leaves the tower ring
NECK_X = 70.0      # X where the neck blend runs into the web face
NECK_ZB = 60.0     # height at which the blend meets the web face at NECK_X
# cylinder (axis along Y) shaping the slanted tower top; tangent to the housing circle
CUT_XC, CUT_ZC = -127.5, 227.5

HX, HZ, HR = 97.0, 100.0, 54.0   # tilt housing axis X, Z (above disk top), radius
HY0, HY1 = -24.0, 23.0           # housing / web Y extent (front face, back face)
BACK_REC_R, BACK_REC_D = 44.0, 4.0   # recess in the housing back face
BACK_HOLE_R = 39.0                   # screw circle on the recess floor

DISC_R, DISC_H = 34.0, 2.5       # raised cover disc on the front face
BOLT_R = 41.0                    # front screw circle radius
FACE_SCREWS = [100, 76, 52, 28, 4, -20, -44, -68]
BAND_SCREWS = [172, 196, 220]
BAND_RI, BAND_RO, BAND_H = 34.0, 46.5, 8.0   # V-band clamp on the front face
BAND_CH = 4.0                    # bevel on the inner edge of the band
BAND_A0, BAND_A1 = 141.0, 259.0  # polar extent of the band (deg, CCW from +X seen from front)
BLOCK_A, BLOCK_H = 19.0, 12.0    # clamp end blocks (angular width deg, height)
BLOCK_R0, BLOCK_R1 = 35.0, 47.5  # radial extent of the end blocks
PILL_W, PILL_H = 7.6, 9.0        # obround bosses on the web face
PILLS = [((48.5, 36.0), (68.6, 56.0)), ((67.6, 21.0), (86.6, 40.0))]

MOT = 57.0         # stepper motor square size
MOT_NOTCH = 9.0    # stepped corner relief of the motor body
MOT_FIL = 2.5      # rounding of the motor section corners
VM_H = 99.0        # vertical motor top above disk top
HM_FL = 9.0        # horizontal motor flange length
HM_FL_W = 56.0     # horizontal motor flange width (along X)
HM_L = 96.5        # horizontal motor length behind housing (incl. flange)
HM_GROOVES = [46.0, 68.0, 90.5]   # groove positions behind housing back face

GROOVE_X0, GROOVE_X1, GROOVE_D = 6.0, 19.0, 1.0   # radial cable grooves at +-Y
RIDGE_RC, RIDGE_RT = 78.0, 13.0                   # curved ramp ridge on the disk
RIDGE_A0, RIDGE_A1 = 104.0, 163.0

Zd = T             # disk top height
HZa = Zd + HZ      # absolute housing axis height
CUT_R = math.hypot(CUT_XC - HX, CUT_ZC - HZ) - HR


def pol(r, a_deg, cx=0.0, cy=0.0):
    a = math.radians(a_deg)
    return (cx + r * math.cos(a), cy + r * math.sin(a))


def motor_section(notch=True):
    """NEMA-like stepper cross-section: square with stepped (notched) corners"""
    h = MOT / 2.0
    sk = cq.Sketch().rect(MOT, MOT)
    if notch:
        sk = sk.push([(h, h), (-h, h), (h, -h), (-h, -h)]).rect(2 * MOT_NOTCH, 2 * MOT_NOTCH, mode="s")
    return sk.reset().vertices().fillet(MOT_FIL)


def motor_body(length, grooves):
    """stepper body along +Z from z=0 with thin lamination grooves"""
    b = cq.Workplane("XY").placeSketch(motor_section()).extrude(length)
    for gz in grooves:
        ring_cut = (cq.Workplane("XY").workplane(offset=gz - 0.5)
                    .rect(MOT + 4, MOT + 4).rect(MOT - 1.6, MOT - 1.6).extrude(1.0))
        b = b.cut(ring_cut)
    return b


def front_wp(dy=0.0):
    """workplane on the housing front face (Y=HY0), extruding towards -Y; local (u,v)=(X,Z)"""
    return cq.Workplane("XZ").workplane(offset=-HY0 + dy)


def housing_revolve(section, a0, a1):
    """revolve a (radius, depth-in-front-of-face) section about the housing axis
    over the polar angles a0..a1 (deg, CCW seen from the front, 0 = +X)"""
    pts = [(r, HY0 - d) for r, d in section]
    w = (cq.Workplane("XY", origin=(HX, 0.0, HZa)).polyline(pts).close()
         .revolve(a1 - a0, (0, 0, 0), (0, 1, 0)))
    return w.rotate((HX, 0.0, HZa), (HX, 1.0, HZa), -a1)


# ---------------- base disk ----------------
disk = cq.Workplane("XY").circle(R).extrude(T)
disk = disk.faces(">Z").edges().chamfer(EDGE_CH)

# ---------------- tower ring + web + tilt housing ----------------
ring = cq.Workplane("XY").workplane(offset=Zd).circle(RING_RO).extrude(200.0)

# tangent point between the shaping cylinder and the housing circle
ang_t = math.atan2(CUT_ZC - HZ, CUT_XC - HX)
PT = (HX + HR * math.cos(ang_t), HZ + HR * math.sin(ang_t))

th1 = math.radians(-12.0)
p_t1 = (HX + HR * math.cos(th1), HZ + HR * math.sin(th1))
web = (
    cq.Workplane("XZ").workplane(offset=-HY1)
    .moveTo(0.0, Zd - 1.0)
    .lineTo(R - 4.0, Zd - 1.0)
    .spline([(R + 19.0, Zd + 21.0), (R + 39.0, Zd + 52.0), (p_t1[0], Zd + p_t1[1])],
            includeCurrent=True)
    .threePointArc((HX, Zd + HZ + HR), (PT[0], Zd + PT[1]))
    .lineTo(0.0, Zd + PT[1])
    .close()
    .extrude(HY1 - HY0)
)

cutter = (cq.Workplane("XZ").workplane(offset=-200.0)
          .center(CUT_XC, Zd + CUT_ZC).circle(CUT_R).extrude(400.0))
# region above the housing circle (right of the tangent point)
a_mid = ang_t / 2.0
cutter2 = (
    cq.Workplane("XZ").workplane(offset=-200.0)
    .moveTo(PT[0], Zd + PT[1])
    .lineTo(PT[0], Zd + 400.0)
    .lineTo(HX + HR + 60.0, Zd + 400.0)
    .lineTo(HX + HR + 60.0, HZa)
    .lineTo(HX + HR, HZa)
    .threePointArc((HX + HR * math.cos(a_mid), HZa + HR * math.sin(a_mid)),
                   (PT[0], Zd + PT[1]))
    .close()
    .extrude(400.0)
)
bore = cq.Workplane("XY").workplane(offset=Zd).circle(RING_RI).extrude(250.0)

# tower ring: slanted top, bore, rounded rim
ring = ring.rotate((0, 0, 0), (0, 0, 1), 180.0)   # keep the cylinder seams away from the housing side
ring = ring.cut(cutter).cut(bore.rotate((0, 0, 0), (0, 0, 1), 180.0))
rim = [e for e in ring.edges().vals() if e.geomType() == "BSPLINE" and e.Center().z > Zd + 20.0]
ring = cq.Workplane("XY").add(ring.val().fillet(RIM_FILLET, rim))
ring = ring.cut(cutter2)

# concave blends (neck) between ring and web faces: spline leaving the ring
# tangentially and running into the flat web face
for yface, sgn in ((HY1, 1.0), (HY0, -1.0)):
    yo = abs(yface)
    a_r = math.radians(NECK_A)
    pr = (RING_RO * math.cos(a_r), RING_RO * math.sin(a_r))
    t_r = (math.sin(a_r), -math.cos(a_r))
    r_in = RING_RO - 6.0
    p_in = (math.sqrt(r_in ** 2 - (yo - 3.0) ** 2), yo - 3.0)
    a_in = math.atan2(p_in[1], p_in[0])
    a_m = (a_in + a_r) / 2.0
    filler = (cq.Workplane("XY").workplane(offset=Zd)
              .moveTo(pr[0], sgn * pr[1])
              .spline([(NECK_X, sgn * yo)], tangents=[(t_r[0], sgn * t_r[1]), (1.0, 0.0)],
                      includeCurrent=True)
              .lineTo(NECK_X, sgn * (yo - 3.0))
              .lineTo(p_in[0], sgn * p_in[1])
              .threePointArc((r_in * math.cos(a_m), sgn * r_in * math.sin(a_m)),
                             (r_in * math.cos(a_r), sgn * r_in * math.sin(a_r)))
              .close()
              .extrude(200.0))
    # the blend dies out towards the top: trim it with a plane through the rim at the
    # ring, the rim at the web face and a low point on the web face
    zf = lambda x: Zd + CUT_ZC - math.sqrt(CUT_R ** 2 - (x - CUT_XC) ** 2)
    pa = cq.Vector(pr[0], sgn * pr[1], zf(pr[0]))
    pc = cq.Vector(PT[0], sgn * yo, Zd + PT[1])
    pb = cq.Vector(NECK_X, sgn * yo, Zd + NECK_ZB)
    nrm = (pc - pa).cross(pb - pa)
    if nrm.z < 0:
        nrm = -nrm
    trim = (cq.Workplane(cq.Plane(origin=pa, xDir=(pc - pa).normalized(), normal=nrm.normalized()))
            .rect(600.0, 600.0).extrude(300.0))
    filler = filler.cut(trim)
    web = web.union(filler)

web = web.cut(cutter).cut(cutter2)
web = web.cut(cq.Workplane("XY").workplane(offset=Zd - 5.0).circle(RING_RO - 6.0).extrude(250.0))

housing = (cq.Workplane("XZ").workplane(offset=-HY1)
           .center(HX, HZa).circle(HR).extrude(HY1 - HY0)).cut(bore)
body = ring.union(web).union(housing)

# ---------------- front face of the housing ----------------
feat = front_wp().center(HX, HZa).circle(DISC_R).extrude(DISC_H)

# V-band clamp (trapezoid section revolved about the housing axis)
band = housing_revolve([(BAND_RI, -0.5), (BAND_RO, -0.5), (BAND_RO, BAND_H),
                        (BAND_RI + BAND_CH, BAND_H), (BAND_RI, BAND_H - BAND_CH)],
                       BAND_A0, BAND_A1)
feat = feat.union(band)

# end blocks (trunnions) at both ends of the band, bolt heads on their free end faces
for a_end, d in ((BAND_A0, -1.0), (BAND_A1, 1.0)):
    a_free = a_end + d * BLOCK_A * 0.5
    a_in = a_end - d * BLOCK_A * 0.5
    blk = housing_revolve([(BLOCK_R0, -0.5), (BLOCK_R1, -0.5), (BLOCK_R1, BLOCK_H - 1.5),
                           (BLOCK_R1 - 1.5, BLOCK_H), (BLOCK_R0, BLOCK_H)],
                          min(a_free, a_in), max(a_free, a_in))
    rc = (BLOCK_R0 + BLOCK_R1) / 2.0
    c = pol(rc, a_free, HX, HZa)
    ar = math.radians(a_free)
    n = cq.Vector(-math.sin(ar) * d, 0.0, math.cos(ar) * d)
    head = (cq.Workplane(cq.Plane(origin=(c[0], HY0 - BLOCK_H / 2.0, c[1]), xDir=(0, 1, 0), normal=n))
            .circle(3.6).extrude(1.6))
    feat = feat.union(blk).union(head)

# screw heads
for a in FACE_SCREWS:
    p = pol(BOLT_R, a, HX, HZa)
    s = front_wp().center(*p).circle(2.7).extrude(2.0)
    s = s.cut(front_wp(1.0).center(*p).circle(1.2).extrude(1.0))
    feat = feat.union(s)
for a in BAND_SCREWS:
    p = pol(BOLT_R + 0.5, a, HX, HZa)
    s = front_wp(BAND_H).center(*p).circle(2.7).extrude(1.5)
    s = s.cut(front_wp(BAND_H + 0.5).center(*p).circle(1.2).extrude(1.0))
    feat = feat.union(s)

# retaining tab on top of the housing front
tab = (cq.Workplane("XZ").workplane(offset=-HY0 - 5.0)
       .polyline([(HX - 8.5, HZa + HR - 6.0), (HX + 8.5, HZa + HR - 6.0),
                  (HX + 6.0, HZa + HR + 8.0), (HX - 6.0, HZa + HR + 8.0)])
       .close().extrude(5.0))
feat = feat.union(tab)

# obround bosses on the web face
for (x0, z0), (x1, z1) in PILLS:
    L = math.hypot(x1 - x0, z1 - z0) - PILL_W
    ang = math.degrees(math.atan2(z1 - z0, x1 - x0))
    pill = (front_wp().center((x0 + x1) / 2.0, Zd + (z0 + z1) / 2.0)
            .transformed(rotate=(0, 0, ang)).slot2D(L + PILL_W, PILL_W).extrude(PILL_H))
    feat = feat.union(pill)

body = body.union(feat)

# back face: shallow recess around the motor adapter
body = body.cut(cq.Workplane("XZ").workplane(offset=-HY1)
                .center(HX, HZa).circle(BACK_REC_R).extrude(BACK_REC_D))
# screw holes on the recess floor around the motor adapter
back_holes = [pol(BACK_HOLE_R, 22.5 + 45.0 * k, HX, HZa) for k in range(8)]
body = body.cut(cq.Workplane("XZ").workplane(offset=-HY1 + BACK_REC_D)
                .pushPoints(back_holes).circle(1.8).extrude(6.0))

# ---------------- join tower to the base disk ----------------
result = disk.union(body)
base_edges = []
for e in result.edges().vals():
    pts = [e.positionAt(t) for t in (0.0, 0.25, 0.5, 0.75, 1.0)]
    if all(abs(p.z - T) < 1e-3 for p in pts) and all(math.hypot(p.x, p.y) > RING_RO - 0.5 for p in pts) \
            and all(math.hypot(p.x, p.y) < R - 3.0 for p in pts):
        base_edges.append(e)
result = cq.Workplane("XY").add(result.val().fillet(BASE_FILLET, base_edges))

# ---------------- base disk details ----------------
r_clear = RING_RO + BASE_FILLET + 0.5
# radial cable grooves at +Y and -Y (running up to the tower)
for sgn in (1, -1):
    g0 = RING_RO - 1.0
    g = (cq.Workplane("XY").workplane(offset=T - GROOVE_D)
         .center((GROOVE_X0 + GROOVE_X1) / 2.0, sgn * (g0 + R + 2.0) / 2.0)
         .rect(GROOVE_X1 - GROOVE_X0, R + 2.0 - g0).extrude(GROOVE_D + BASE_FILLET + 1.0))
    result = result.cut(g)
# flat pad at -X on top, notch underneath
pad = (cq.Workplane("XY").workplane(offset=T - 0.8)
       .polyline([(-R - 2, -17.0), (-r_clear, -15.0), (-r_clear, 17.0), (-R - 2, 21.0)])
       .close().extrude(2.0))
result = result.cut(pad)
result = result.cut(cq.Workplane("XY").center(-R + 21.0, 0.0).rect(44.0, 23.0).extrude(1.5))

# curved ramp ridge (tilted torus segment sinking into the disk)
beta = (RIDGE_A0 + RIDGE_A1) / 2.0
half = math.radians((RIDGE_A1 - RIDGE_A0) / 2.0)
z_hi, z_lo = T + 3.0, T - RIDGE_RT - 1.0
alpha = math.degrees((z_hi - z_lo) / (2.0 * RIDGE_RC * math.sin(half)))
h0 = (z_hi + z_lo) / 2.0
ridge = (cq.Workplane("XZ").center(RIDGE_RC, h0).circle(RIDGE_RT)
         .revolve(RIDGE_A1 - RIDGE_A0, (-RIDGE_RC, 0, 0), (-RIDGE_RC, 1, 0)))
ridge = ridge.rotate((0, 0, 0), (0, 0, 1), RIDGE_A0)
ridge = ridge.rotate((0, 0, 0), (math.cos(math.radians(beta)), math.sin(math.radians(beta)), 0), alpha)
ridge = ridge.intersect(cq.Workplane("XY").rect(4 * R, 4 * R).extrude(60.0))
result = result.union(ridge)

# ---------------- vertical (pan) motor inside the tower ----------------
vmot = motor_body(VM_H, [VM_H - 8.0, VM_H - 31.0, VM_H - 54.0]).translate((0, 0, Zd))
vmot = vmot.union(cq.Workplane("XY").workplane(offset=Zd + VM_H).circle(7.6).extrude(4.0))
result = result.union(vmot)

# ---------------- horizontal (tilt) motor behind the housing ----------------
body_len = HM_L - HM_FL
hm = motor_body(body_len, [g - HM_FL for g in HM_GROOVES])
hm = hm.union(cq.Workplane("XY").workplane(offset=body_len).circle(7.3).extrude(4.5))
hm = hm.translate((0, 0, HM_FL))
fl = cq.Workplane("XY").workplane(offset=-4.0).rect(HM_FL_W, MOT - 1.0).extrude(HM_FL + 4.0)
hm = hm.union(fl.edges("|Z").fillet(3.0))
# motor axis along +Y starting at the housing back face
hm = hm.rotate((0, 0, 0), (1, 0, 0), -90).translate((HX, HY1, HZa))
result = result.union(hm)
